import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Quad frame plate: flat base plate with four round mounting tabs, an
# irregular curvy-diamond central window, a thinner raised rail layer on top
# (inset by a small ledge on every edge), tapered rail strips on the arms that
# end in ramps short of the tabs, and a small thorn-shaped locating notch on
# the -X side of the window.
# Planform dimensions are in "u" planform units; UNIT converts u to mm.
# ---------------------------------------------------------------------------
UNIT = 0.5                 # mm per planform unit
HOLE_PITCH_X = 196.6       # hole centre spacing along X (u)
HOLE_PITCH_Y = 196.4       # hole centre spacing along Y (u)
TAB_R = 20.3               # tab outer radius (u)
HOLE_R = 7.9               # mounting hole radius (u)
T_BASE = 6.9               # base plate thickness (u)
T_RAIL = 4.4               # raised rail thickness (u)
LEDGE_OUT = 1.5            # rail inset from the outer edges (u)
LEDGE_IN = 1.8             # rail set-back from the window edge (u)
RAMP_RUN = 12.0            # horizontal run of the rail end ramps (u)
RAMP_FOOT_SLOPE = 0.2      # ramp slope where it meets the tab surface
WIN_FILLETS = [8.0, 3.3, 4.1, 4.3]        # window corner radii  UL, LL, LR, UR (u)
RAIL_WIN_FILLETS = [8.6, 5.1, 5.9, 6.1]   # rail window corner radii (u)

HX, HY = HOLE_PITCH_X / 2.0, HOLE_PITCH_Y / 2.0
TABS = {"UR": (HX, HY), "UL": (-HX, HY), "LL": (-HX, -HY), "LR": (HX, -HY)}

# Outer edge of each bay between two tabs, listed CCW, as a tangent arc chain:
#  tab A -> concave fillet rhoA -> concave bay arc (centre, R) -> concave fillet rhoB -> tab B
BAYS = [
    ("UR", "UL", (-0.74, 133.70), 86.00, 72.20, 76.04),
    ("UL", "LL", (-163.31, 0.76), 98.31, 77.18, 92.15),
    ("LL", "LR", (-14.93, -133.30), 98.85, 55.63, 89.11),
    ("LR", "UR", (132.52, 0.02), 84.74, 61.33, 42.26),
]

# Window boundary arcs (the window lies outside these discs), CCW order.
WIN_ARCS = {
    "top": ((0.14, 138.00), 97.58),
    "left": ((-157.95, -1.02), 101.96),
    "bottom": ((-15.00, -140.13), 113.46),
    "right": ((148.61, 0.50), 109.04),
}

# Rail strips on the arms: tab, (end corner A, edge line A), (end corner B, edge line B)
STRIPS = [
    ("UR", (86.4, 90.6), [(73.2, 81.1), (63.9, 73.1), (54.7, 66.3)],
           (91.1, 86.5), [(82.4, 77.4), (75.5, 69.6), (69.7, 61.5), (63.9, 53.4), (59.5, 45.5)]),
    ("UL", (-86.2, 88.6), [(-79.9, 83.1), (-73.7, 80.0), (-67.6, 76.9), (-62.2, 73.1), (-59.1, 70.0)],
           (-91.4, 83.4), [(-85.1, 70.8), (-81.1, 56.9), (-78.2, 50.0)]),
    ("LL", (-94.3, -83.9), [(-88.7, -72.7), (-84.0, -62.0), (-80.0, -52.0)],
           (-88.6, -86.7), [(-83.6, -78.5), (-76.6, -66.9), (-69.1, -55.4), (-64.0, -50.0)]),
    ("LR", (84.7, -89.6), [(73.2, -79.2), (61.6, -68.9), (55.0, -63.0)],
           (89.9, -85.0), [(83.6, -75.8), (73.2, -64.2), (60.5, -49.2), (56.5, -41.0)]),
]

# Thorn-shaped locating notch on the -X window edge (base height only)
NOTCH_TIP = (-41.4, -0.2)
NOTCH_HALF = 8.6           # half width of the notch root along the window edge (u)
NOTCH_SAG = 1.2            # concavity (sagitta) of the notch flanks (u)


# ------------------------------- helpers -----------------------------------
def V(p, z=0.0):
    return cq.Vector(p[0] * UNIT, p[1] * UNIT, z * UNIT)


def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def add(a, b, s=1.0):
    return (a[0] + s * b[0], a[1] + s * b[1])


def sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def on_circle(c, r, ang_deg):
    a = math.radians(ang_deg)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def ang_of(c, p):
    return math.degrees(math.atan2(p[1] - c[1], p[0] - c[0]))


def circ_inter(c1, r1, c2, r2, near):
    d = math.hypot(c2[0] - c1[0], c2[1] - c1[1])
    a = (r1 * r1 - r2 * r2 + d * d) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    m = (c1[0] + a * (c2[0] - c1[0]) / d, c1[1] + a * (c2[1] - c1[1]) / d)
    n = (-(c2[1] - c1[1]) / d, (c2[0] - c1[0]) / d)
    s1, s2 = add(m, n, h), add(m, n, -h)
    return s1 if math.hypot(*sub(s1, near)) < math.hypot(*sub(s2, near)) else s2


def arc_edge(c, r, p0, p1):
    """Shorter circular arc from p0 to p1 about centre c."""
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    da = (a1 - a0 + math.pi) % (2 * math.pi) - math.pi
    pm = (c[0] + r * math.cos(a0 + da / 2), c[1] + r * math.sin(a0 + da / 2))
    return cq.Edge.makeThreePointArc(V(p0), V(pm), V(p1))


# --------------------------- outer boundary --------------------------------
def bay_edges(bay, inset):
    """Edges of one bay (tab A departure -> tab B arrival) and the two tab angles."""
    rt = TAB_R - inset
    ta, tb, cb, rb, rho_a, rho_b = bay
    ca, cbb = TABS[ta], TABS[tb]
    # fillet centres: tangent to the tab circle (outside) and the bay circle (inside)
    fa = circ_inter(ca, TAB_R + rho_a, cb, rb - rho_a, cbb)
    fb = circ_inter(cbb, TAB_R + rho_b, cb, rb - rho_b, ca)
    rb_i, ra_i, rbb_i = rb + inset, rho_a + inset, rho_b + inset
    ta0 = add(ca, unit(sub(fa, ca)), rt)
    ta1 = add(cb, unit(sub(fa, cb)), rb_i)
    tb1 = add(cb, unit(sub(fb, cb)), rb_i)
    tb0 = add(cbb, unit(sub(fb, cbb)), rt)
    edges = [arc_edge(fa, ra_i, ta0, ta1), arc_edge(cb, rb_i, ta1, tb1),
             arc_edge(fb, rbb_i, tb1, tb0)]
    return edges, ta, ang_of(ca, fa), tb, ang_of(cbb, fb)


def outline_wire(inset=0.0):
    """Closed CCW outer boundary; inset > 0 gives the boundary offset inwards."""
    parts = [bay_edges(b, inset) for b in BAYS]
    edges = []
    n = len(parts)
    for i in range(n):
        e, ta, aa, tb, ab = parts[i]
        edges += e
        nxt = parts[(i + 1) % n]
        start, end = ab, nxt[2]
        while end <= start:
            end += 360.0
        c, r = TABS[tb], TAB_R - inset
        edges.append(cq.Edge.makeThreePointArc(V(on_circle(c, r, start)),
                                               V(on_circle(c, r, 0.5 * (start + end))),
                                               V(on_circle(c, r, end))))
    return cq.Wire.assembleEdges(edges)


# ------------------------------ window -------------------------------------
def window_wire(shrink, fillets):
    order = ["top", "left", "bottom", "right"]
    circles = {k: (WIN_ARCS[k][0], WIN_ARCS[k][1] - shrink) for k in order}
    corners = []
    for i in range(4):
        (ca, ra), (cb, rb) = circles[order[i]], circles[order[(i + 1) % 4]]
        rf = fillets[i]
        f = circ_inter(ca, ra + rf, cb, rb + rf, (0.0, 0.0))
        corners.append((f, add(ca, unit(sub(f, ca)), ra), add(cb, unit(sub(f, cb)), rb), rf))
    edges = []
    for i in range(4):
        f, ta, tb, rf = corners[i]
        edges.append(arc_edge(f, rf, ta, tb))
        cb, rb = circles[order[(i + 1) % 4]]
        edges.append(arc_edge(cb, rb, tb, corners[(i + 1) % 4][1]))
    return cq.Wire.assembleEdges(edges)


def prism(wire, z0, h):
    face = cq.Face.makeFromWires(wire)
    sol = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, h * UNIT))
    return cq.Workplane("XY").add(sol.translate(cq.Vector(0, 0, z0 * UNIT)))


# ------------------------------ base plate ---------------------------------
outer = outline_wire()
base = prism(outer, 0, T_BASE)
base = base.cut(prism(window_wire(0.0, WIN_FILLETS), -1, T_BASE + T_RAIL + 2))
for c in TABS.values():
    base = base.cut(cq.Workplane("XY").center(c[0] * UNIT, c[1] * UNIT)
                    .circle(HOLE_R * UNIT).extrude((T_BASE + 2) * UNIT)
                    .translate((0, 0, -UNIT)))

# thorn notch: slightly concave flanks from the window edge to a sharp tip
wc, wr = WIN_ARCS["left"]
def edge_pt(y):
    return (wc[0] + math.sqrt(wr * wr - (y - wc[1]) ** 2), y)
def flank_mid(p, q):
    """Mid point of p->q pulled NOTCH_SAG towards the notch axis (concave flank)."""
    m = add(p, sub(q, p), 0.5)
    n = unit((-(q[1] - p[1]), q[0] - p[0]))
    if (NOTCH_TIP[1] - m[1]) * n[1] < 0:
        n = (-n[0], -n[1])
    return add(m, n, NOTCH_SAG)
r0 = edge_pt(NOTCH_TIP[1] + NOTCH_HALF)
r1 = edge_pt(NOTCH_TIP[1] - NOTCH_HALF)
back = 4.0
notch_w = cq.Wire.assembleEdges([
    cq.Edge.makeThreePointArc(V(r0), V(flank_mid(r0, NOTCH_TIP)), V(NOTCH_TIP)),
    cq.Edge.makeThreePointArc(V(NOTCH_TIP), V(flank_mid(r1, NOTCH_TIP)), V(r1)),
    cq.Edge.makeLine(V(r1), V((r1[0] - back, r1[1]))),
    cq.Edge.makeLine(V((r1[0] - back, r1[1])), V((r0[0] - back, r0[1]))),
    cq.Edge.makeLine(V((r0[0] - back, r0[1])), V(r0)),
])
base = base.union(prism(notch_w, 0, T_BASE))

# ------------------------------ raised rail --------------------------------
rail = prism(outline_wire(LEDGE_OUT), T_BASE, T_RAIL)
rail = rail.cut(prism(window_wire(LEDGE_IN, RAIL_WIN_FILLETS), T_BASE - 1, T_RAIL + 2))

for tab, end_a, line_a, end_b, line_b in STRIPS:
    tc = TABS[tab]
    d = unit(tc)
    pa = unit(sub(line_a[-1], line_b[-1]))
    pb = (-pa[0], -pa[1])
    la, lb = line_a[-1], line_b[-1]
    loop = [add(la, pa, 30), add(add(tc, d, 50), pa, 50), add(add(tc, d, 50), pb, 50), add(lb, pb, 30)]
    edges = [cq.Edge.makeSpline([V(p) for p in [end_a] + line_a])]
    pts = [la] + loop + [lb]
    for k in range(len(pts) - 1):
        edges.append(cq.Edge.makeLine(V(pts[k]), V(pts[k + 1])))
    edges.append(cq.Edge.makeSpline([V(p) for p in list(reversed(line_b)) + [end_b]]))
    edges.append(cq.Edge.makeLine(V(end_b), V(end_a)))
    rail = rail.cut(prism(cq.Wire.assembleEdges(edges), T_BASE - 1, T_RAIL + 2))
    # ramp rising from the strip end toward the frame centre
    e = ((end_a[0] + end_b[0]) / 2, (end_a[1] + end_b[1]) / 2)
    u = unit(sub(end_b, end_a))
    dd = (-u[1], u[0])
    if dd[0] * d[0] + dd[1] * d[1] < 0:
        dd = (-dd[0], -dd[1])
    pl = cq.Plane(origin=V(e), xDir=cq.Vector(dd[0], dd[1], 0),
                  normal=cq.Vector(dd[1], -dd[0], 0))
    z_top, z_bot = (T_BASE + T_RAIL) * UNIT, T_BASE * UNIT
    foot = unit((1.0, -RAMP_FOOT_SLOPE))
    cutter = (cq.Workplane(pl)
              .moveTo(-RAMP_RUN * UNIT, z_top)
              .spline([(0, z_bot)], tangents=[(1, 0), foot], includeCurrent=True)
              .lineTo(0.5 * UNIT, z_bot - UNIT)
              .lineTo(60 * UNIT, z_bot - UNIT)
              .lineTo(60 * UNIT, z_top + 5 * UNIT)
              .lineTo(-RAMP_RUN * UNIT, z_top + 5 * UNIT)
              .close()
              .extrude(30 * UNIT, both=True))
    rail = rail.cut(cutter)

result = base.union(rail)
